import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 100.0            # plate size (square) and overall depth (front to back)
T = 4.0              # plate thickness
R_NECK = 10.0        # strut radius in the middle
R_FRONT = 12.5       # strut radius where it meets the front plate
FRONT_FLARE = 7.5    # length of the front flare
R_BELL = 31.0        # bell radius where it meets the back plate
BELL_LEN = 32.0      # length of the back bell (trumpet)
SEC_T = 1.12         # section stretch, tangential (around the part axis)
SEC_R = 0.85         # section stretch, radial (towards the part axis)
# strut centre-line positions (|x|, |z|) at the front and back inner plate faces
AX_F, AZ_F = 36.8, 37.9
AX_B, AZ_B = 26.0, 26.5
# small dimples on the outer flanks of each bell
DIMPLE_Y = 40.5      # Y position of the dimples
DIMPLE_R = 3.4       # dimple mouth radius
DIMPLE_DEPTH = 3.5   # dimple depth below the bell surface
DIMPLE_TAPER = 22.0  # wall taper of the dimples (deg)

Y_IN = L / 2 - T     # inner faces of the plates at +-Y_IN
EXT = 1.5            # strut extension into the plates


def unit(x, y):
    ln = math.hypot(x, y)
    return (x / ln, y / ln)


def strut(sx, sz):
    """Strut between the plates.

    Built as a solid of revolution about the Y axis (front flare, slender
    neck, trumpet bell) and then sheared so that its centre line runs from
    the front corner region towards the middle of the back plate while every
    cross-section stays parallel to the plates.
    """
    y0, y1 = -Y_IN, Y_IN
    fl, bl = FRONT_FLARE, BELL_LEN
    # (r, y) profile points of the outer contour
    pts = [
        (R_NECK + 0.55 * (R_FRONT - R_NECK), y0 + 0.28 * fl),
        (R_NECK + 0.15 * (R_FRONT - R_NECK), y0 + 0.65 * fl),
        (R_NECK, y0 + fl + 6.0),
        (R_NECK - 0.2, y0 + fl + 6.0 + 0.3 * (y1 - bl - y0 - fl - 6.0)),
        (R_NECK - 0.2, y0 + fl + 6.0 + 0.7 * (y1 - bl - y0 - fl - 6.0)),
        (R_NECK + 0.1, y1 - bl),
        (R_NECK + 2.5, y1 - 0.53 * bl),
        (R_NECK + 5.0, y1 - 0.25 * bl),
        (R_NECK + 8.0, y1 - 0.13 * bl),
        (R_NECK + 12.0, y1 - 0.047 * bl),
        (R_BELL, y1),
    ]
    prof = (
        cq.Workplane("XY")
        .moveTo(0, y0 - EXT)
        .lineTo(R_FRONT, y0 - EXT)
        .lineTo(R_FRONT, y0)
        .spline(pts, tangents=[unit(-1.0, 1.1), unit(1.0, 0.12)],
                includeCurrent=True, scale=False)
        .lineTo(R_BELL, y1 + EXT)
        .lineTo(0, y1 + EXT)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
    )
    solid = prof.val()
    # put the revolution seam on the hidden inner side
    solid = solid.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0),
                         math.degrees(math.atan2(sz, -sx)))
    # slightly flattened section (thinner radially than tangentially),
    # shear + move: centre line from the front corner region towards the
    # middle of the back plate, cross-sections stay parallel to the plates
    kx = sx * (AX_B - AX_F) / (y1 - y0)
    kz = sz * (AZ_B - AZ_F) / (y1 - y0)
    tx = sx * 0.5 * (AX_F + AX_B)
    tz = sz * 0.5 * (AZ_F + AZ_B)
    a11 = 0.5 * (SEC_T + SEC_R)
    a13 = 0.5 * sx * sz * (SEC_R - SEC_T)
    m = cq.Matrix([[a11, kx, a13, tx],
                   [0.0, 1.0, 0.0, 0.0],
                   [a13, kz, a11, tz]])
    return solid.transformGeometry(m)


# four struts
body = None
for sx in (-1, 1):
    for sz in (-1, 1):
        st = cq.Workplane("XY").newObject([strut(sx, sz)])
        body = st if body is None else body.union(st)

# the bells spread to the plate edges: trim them flush with the plate outline
clip = cq.Workplane("XY").box(L, 2 * (Y_IN + EXT), L)
body = body.intersect(clip)

front = cq.Workplane("XY").box(L, T, L).translate((0, -(L / 2 - T / 2), 0))
back = cq.Workplane("XY").box(L, T, L).translate((0, (L / 2 - T / 2), 0))
result = body.union(front).union(back)


# ---------------- dimples on the outer flanks of the bells ----------------
def surface_point(solid, start, direction, length=30.0, step=0.7):
    """First point where the ray start + t*direction enters the solid."""
    lo, hi = 0.0, None
    for i in range(1, int(length / step) + 1):
        t = step * i
        if solid.isInside(start + direction * t):
            hi = t
            break
        lo = t
    if hi is None:
        return None
    for _ in range(16):
        mid = 0.5 * (lo + hi)
        if solid.isInside(start + direction * mid):
            hi = mid
        else:
            lo = mid
    return start + direction * hi


solid = result.val()
cutters = []
for sx in (-1, 1):
    for sz in (-1, 1):
        t = (DIMPLE_Y + Y_IN) / (2 * Y_IN)
        axx = sx * (AX_F + (AX_B - AX_F) * t)
        azz = sz * (AZ_F + (AZ_B - AZ_F) * t)
        for dirv, start in (
            (cq.Vector(-sx, 0, 0), cq.Vector(sx * (L / 2 + 1.13), DIMPLE_Y, azz)),
            (cq.Vector(0, 0, -sz), cq.Vector(axx, DIMPLE_Y, sz * (L / 2 + 1.13))),
        ):
            p = surface_point(solid, start, dirv)
            if p is None:
                continue
            top = p - dirv * 2.0
            # small tapered triangular pit, apex of the triangle towards the front
            pit = (
                cq.Workplane(cq.Plane(origin=top, xDir=cq.Vector(0, -1, 0),
                                      normal=dirv))
                .polygon(3, 2.0 * DIMPLE_R * 1.55)
                .extrude(2.0 + DIMPLE_DEPTH, taper=DIMPLE_TAPER)
                .val()
            )
            cutters.append(pit)

for c in cutters:
    result = result.cut(cq.Workplane("XY").newObject([c]))

VIEW = {"azimuth": 45, "elevation": 26}
